import math
import cadquery as cq

# =====================================================================
#  Parrot stencil: a thin base plate with parrot-shaped openings (wing, tail,
#  chest slit, talon) and a raised parrot-body layer bonded on top of it.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 250.0          # plate width  (X)
D = 300.0          # plate depth  (Y)
T = 1.5            # plate thickness
H2 = 2 * T         # top of the raised parrot-body layer
NOTCH_X0, NOTCH_X1, NOTCH_D = -39.0, -14.0, 6.0   # notch in the front edge
STRIP_W = 2.6      # width of the feather bands (plate level)
SLOT_W = 0.8       # width of the slit running inside each feather band
BAR_W = 1.6        # width of the bar carrying the lower wing feathers

# ---------------- 2D helpers ----------------
V = lambda p: cq.Vector(p[0], p[1], 0)


def outline(segs):
    """closed face from chained segments; 2-point segment = line, else spline"""
    edges = []
    for pts in segs:
        if len(pts) == 2:
            edges.append(cq.Edge.makeLine(V(pts[0]), V(pts[1])))
        else:
            edges.append(cq.Edge.makeSpline([V(p) for p in pts]))
    return cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))


def polyline_segs(pts):
    return [[pts[i], pts[i + 1]] for i in range(len(pts) - 1)]


def rect_face(x0, y0, x1, y1):
    return outline(polyline_segs([(x0, y0), (x1, y0), (x1, y1), (x0, y1), (x0, y0)]))


def slot_face(p0, p1, width):
    (x0, y0), (x1, y1) = p0, p1
    L = math.hypot(x1 - x0, y1 - y0)
    ang = math.degrees(math.atan2(y1 - y0, x1 - x0))
    w = (cq.Workplane("XY").center((x0 + x1) / 2, (y0 + y1) / 2)
         .slot2D(L + width, width, angle=ang).wires().val())
    return cq.Face.makeFromWires(w)


def strip_face(pts, width):
    """meandering band: chain of straight bands with round joints"""
    faces = [slot_face(a, b, width) for a, b in zip(pts[:-1], pts[1:])]
    f = faces[0]
    if len(faces) > 1:
        f = f.fuse(*faces[1:]).clean()
    return f


def trim(pts, d):
    """shorten an open polyline by d at both ends"""
    def cut_start(p):
        (x0, y0), (x1, y1) = p[0], p[1]
        L = math.hypot(x1 - x0, y1 - y0)
        t = min(d / L, 0.9)
        return [(x0 + t * (x1 - x0), y0 + t * (y1 - y0))] + p[1:]
    p = cut_start(list(pts))
    return cut_start(p[::-1])[::-1]


def ring_face(pts, width, slot):
    """hollow feather band: outer band minus a narrower inner slit"""
    return strip_face(pts, width).cut(strip_face(trim(pts, width), slot)).clean()


def circle_face(x, y, r):
    return cq.Face.makeFromWires(cq.Wire.makeCircle(r, cq.Vector(x, y, 0), cq.Vector(0, 0, 1)))


def extrude(shape, h):
    return [cq.Solid.extrudeLinear(f, cq.Vector(0, 0, h)) for f in shape.Faces()]


# ---------------- outline of the raised body insert ----------------
HEAD = [(-16.4, 61.5), (-24.5, 62.4), (-36.5, 77.5), (-33.5, 126.5), (3.0, 145.0),
        (20.0, 147.5), (66.0, 133.5), (73.0, 68.5), (57.0, 65.0)]
# right flank runs along the middle of the chest slit
SLIT_MID = [(57.0, 65.0), (58.5, 58.0), (59.8, 53.5), (63.5, 46.0), (66.2, 40.0),
            (66.3, 33.0), (65.2, 26.0), (63.0, 20.0), (59.3, 16.5), (57.3, 10.0), (56.0, 4.5),
            (54.0, -3.0), (51.2, -10.0), (48.7, -17.0), (46.7, -24.0), (46.0, -29.0),
            (48.5, -33.0), (51.3, -36.7)]
BODY_R = [(51.3, -36.7), (51.3, -57.3), (48.4, -58.3), (41.2, -58.6)]
CLAW_MID = [(41.2, -58.6), (44.0, -66.0), (40.5, -73.0), (34.0, -76.5), (29.5, -76.5),
            (27.2, -77.5)]
BODY_B = [(27.2, -77.5), (27.0, -99.5), (-11.5, -100.0), (-17.5, -87.0)]
# left flank runs through the inside of the wing / tail opening
BODY_L = [(-17.5, -87.0), (-20.5, -84.0), (-24.0, -82.0), (-28.0, -78.0), (-32.0, -65.0),
          (-38.0, -50.0), (-39.0, -38.0), (-35.0, -24.0), (-25.0, -10.0), (-15.0, 3.0),
          (-8.0, 18.0), (-4.0, 35.0), (-3.0, 52.0), (-10.0, 58.5), (-16.4, 61.5)]

body_outline = outline(polyline_segs(HEAD) + [SLIT_MID] + polyline_segs(BODY_R)
                       + [CLAW_MID] + polyline_segs(BODY_B) + [BODY_L])

# ---------------- through openings ----------------
# wing + tail opening (teardrop wing running into the long tail)
WING = outline([
    [(-21.0, 59.2), (-16.4, 61.5)],
    [(-16.4, 61.5), (-8.0, 64.0), (-2.0, 65.6), (2.7, 65.3), (5.5, 61.0), (6.5, 52.0),
     (6.0, 42.0), (4.5, 33.0), (1.5, 24.0), (-3.0, 13.0), (-9.0, 1.0), (-16.0, -10.0),
     (-22.5, -17.5), (-27.5, -23.0), (-30.5, -31.0), (-31.5, -40.0), (-30.5, -49.0),
     (-28.5, -55.0), (-25.5, -58.5)],
    [(-25.5, -58.5), (-25.0, -63.0), (-24.0, -69.0), (-21.8, -74.3), (-24.6, -78.0),
     (-23.0, -82.5), (-20.8, -84.3)],
    [(-20.8, -84.3), (-24.5, -85.6), (-28.5, -86.3), (-32.0, -86.8), (-33.0, -89.0),
     (-31.8, -92.5), (-31.0, -96.0), (-33.5, -103.0), (-37.9, -110.8), (-42.2, -122.8),
     (-44.5, -134.0), (-45.5, -140.5)],
    [(-45.5, -140.5), (-47.5, -139.0), (-47.8, -126.5), (-47.2, -110.0), (-46.0, -93.0),
     (-45.3, -78.0), (-45.5, -64.0), (-46.4, -50.0), (-47.5, -39.0), (-48.8, -29.0),
     (-49.3, -19.0), (-48.0, -8.0), (-45.5, 1.7), (-41.5, 17.0), (-37.5, 31.0),
     (-33.5, 43.0), (-28.0, 53.5), (-24.5, 57.2), (-21.0, 59.2)],
])

# small detached feather tip beside the tail
TAIL_TIP = slot_face((-51.5, -124.5), (-49.2, -117.0), 2.4)

# narrow chest slit between the body insert and the plate
SLIT = outline([
    [(57.0, 65.3), (57.6, 58.0), (58.3, 53.5), (61.5, 46.0), (63.8, 40.3), (64.0, 33.0),
     (62.5, 26.0), (59.5, 20.5)],
    [(59.5, 20.5), (54.0, 16.5)],
    [(54.0, 16.5), (52.2, 10.0), (51.3, 4.5), (49.5, -3.0), (47.3, -10.1), (45.5, -17.0),
     (44.0, -24.0), (44.2, -29.0), (46.5, -31.0)],
    [(46.5, -31.0), (47.8, -29.0), (49.5, -24.0), (52.0, -17.0), (55.0, -10.0),
     (57.8, -5.8), (60.5, 3.0), (62.5, 10.0), (64.3, 15.6), (67.0, 20.4), (68.6, 30.0),
     (68.7, 39.1), (65.5, 47.0), (60.8, 54.4), (58.3, 61.0), (57.0, 65.3)],
])
# feather loop left standing inside the chest slit (hangs from the plate edge)
SLIT_LOOP = [(57.6, -7.5), (54.8, -2.0), (56.3, 4.0), (57.6, 11.0)]

# talon-shaped opening of the foot
CLAW = outline([
    [(41.2, -58.6), (39.3, -64.0), (37.5, -70.5), (36.2, -74.6)],
    [(36.2, -74.6), (33.3, -73.6), (30.3, -74.0), (28.0, -74.5)],
    [(28.0, -74.5), (27.6, -76.5), (28.5, -79.5), (30.5, -82.0), (35.6, -84.5),
     (43.0, -86.3), (48.5, -87.8), (52.0, -90.2), (53.0, -93.5), (52.0, -97.5)],
    [(52.0, -97.5), (56.0, -101.5), (63.0, -112.5), (68.6, -126.1), (72.3, -130.8)],
    [(72.3, -130.8), (73.8, -127.5), (71.5, -117.0), (66.7, -106.0), (61.5, -96.5)],
    [(61.5, -96.5), (57.0, -87.3)],
    [(57.0, -87.3), (63.5, -93.0)],
    [(63.5, -93.0), (65.7, -92.3)],
    [(65.7, -92.3), (62.0, -85.8), (55.7, -76.7), (48.4, -67.5), (44.5, -62.5),
     (41.2, -58.6)],
])
# round knuckle of the foot, standing at plate level in front of the insert edge
KNOB = (33.5, -75.9, 2.5)

OPENINGS = [WING, SLIT, CLAW, TAIL_TIP]

# ---------------- feather strips left standing inside the wing / tail ----------------
FEATHER_UP = [(-37.5, 38.0), (-31.5, 39.4), (-34.2, 23.7), (-29.2, 14.8), (-19.2, 26.0),
              (-14.0, 27.1), (-15.8, 13.6), (-7.5, 23.7), (-2.8, 22.4), (1.5, 17.0)]
FEATHER_UP_B = [(-29.2, 14.8), (-25.7, 33.0)]
# lower wing: a bar carrying three hanging feather loops
FEATHER_BAR = [(-49.0, 2.5), (-38.6, 6.0), (-29.4, 0.5), (-22.0, -3.5), (-12.0, -9.0)]
FEATHER_LOOPS = [[(-38.6, 6.0), (-41.5, -18.2)],
                 [(-29.4, 0.5), (-32.3, -19.1)],
                 [(-22.0, -3.5), (-24.9, -18.2)]]
# long tail feathers
TAIL_1 = [(-41.5, -18.0), (-41.0, -40.0), (-40.5, -63.6), (-44.2, -92.8), (-46.6, -120.0),
          (-47.0, -134.0)]
TAIL_2 = [(-28.5, -22.0), (-31.7, -26.0), (-33.0, -40.0), (-34.7, -51.4), (-39.8, -61.0)]

strips = ring_face(FEATHER_UP, STRIP_W, SLOT_W).fuse(
    ring_face(FEATHER_UP_B, STRIP_W, SLOT_W), strip_face(FEATHER_BAR, BAR_W),
    *[ring_face(p, STRIP_W, SLOT_W) for p in FEATHER_LOOPS],
    ring_face(TAIL_1, STRIP_W, SLOT_W), ring_face(TAIL_2, STRIP_W, SLOT_W)).clean()
slit_loop = ring_face(SLIT_LOOP, 3.0, SLOT_W)


# ---------------- raised body layer (2D) ----------------
body2d = body_outline.cut(*OPENINGS)

# the base plate has an opening underneath the insert; the insert's top layer
# overlaps its rim all round (wide rim around the head, narrow along the openings)
RECESS = outline([
    [(-19.7, 67.2), (-21.6, 72.7)], [(-21.6, 72.7), (-17.9, 127.1)],
    [(-17.9, 127.1), (17.2, 138.5)], [(17.2, 138.5), (50.7, 128.2)],
    [(50.7, 128.2), (53.8, 67.1)],
    [(53.8, 67.1), (54.5, 58.0), (55.5, 52.0), (58.3, 45.5), (60.6, 40.0), (60.8, 33.0),
     (59.3, 27.0), (56.5, 22.5), (51.5, 15.0), (49.2, 9.5), (48.3, 4.0), (46.5, -3.5),
     (44.3, -10.5), (42.5, -17.5), (41.0, -24.0), (40.3, -30.0), (41.0, -40.0),
     (41.0, -49.5), (37.2, -55.0), (31.1, -69.0), (22.2, -72.6)],
    [(22.2, -72.6), (7.4, -76.0), (-17.3, -75.0)],
    [(-17.3, -75.0), (-21.0, -69.0), (-22.0, -63.0), (-23.0, -58.0), (-25.5, -55.0),
     (-27.5, -49.0), (-28.5, -40.0), (-27.5, -31.0), (-24.8, -23.0), (-20.0, -17.5),
     (-13.5, -10.0), (-6.3, 1.0), (-0.2, 13.0), (4.3, 24.0), (7.3, 33.0), (9.0, 42.0),
     (9.5, 52.0), (8.5, 61.0), (5.5, 66.5), (0.0, 68.5), (-8.0, 67.0), (-16.0, 64.5),
     (-19.7, 67.2)],
])
recess2d = RECESS.intersect(body2d)

# ---------------- base plate (2D) ----------------
plate2d = rect_face(-W / 2, -D / 2, W / 2, D / 2)
notch = rect_face(NOTCH_X0, -D / 2 - 1, NOTCH_X1, -D / 2 + NOTCH_D)
wing_open = WING.cut(strips)          # wing opening with the feather strips left standing
slit_open = SLIT.cut(slit_loop)       # chest slit with its feather loop left standing
plate2d = plate2d.cut(notch, slit_open, CLAW, TAIL_TIP, wing_open)
plate2d = plate2d.fuse(circle_face(*KNOB)).cut(recess2d).clean()

# ---------------- solid: base plate + insert layer on top ----------------
plate = extrude(plate2d, T)
layer = [s.translate(cq.Vector(0, 0, T)) for s in extrude(body2d, H2 - T)]
part = plate[0].fuse(*(plate[1:] + layer)).clean()
result = cq.Workplane("XY").newObject([part])

VIEW = {"azimuth": 45, "elevation": 26}
